import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions.  The layout is drafted on a grid of "units" (u, v) taken
# from the plan view (u to the right = +X, v downwards = -Y) and scaled to mm.
# ---------------------------------------------------------------------------
UNIT = 0.25            # mm per drafting unit
U0, V0 = 130.0, 390.0  # drafting origin

H_PLATE = 35.6 * UNIT   # top of the fan plate / triangle plate
H_RIB = 46.5 * UNIT     # top of the toothed arc rib
H_PIN = 55.0 * UNIT     # top of the two pins
H_TALL = 109.7 * UNIT   # top of the extruded clip profile

PIN_R = 12.5 * UNIT
PIN_CHAMFER = 2.5 * UNIT
PIN1 = (86.5, 367.0)    # pin on the left wing
PIN2 = (135.3, 486.0)   # pin on the lower lobe

TRI_HOLE = (166.1, 369.3)
TRI_HOLE_R = 7.2 * UNIT
TRI_HOLE_CSK = 1.5 * UNIT
BOTTOM_CHAMFER = 1.0 * UNIT

# slit on the underside of the lower lobe
SLIT_U0, SLIT_U1, SLIT_V = 124.0, 150.0, 458.0
SLIT_W = 1.5 * UNIT
SLIT_H = 9.5 * UNIT

BOSS_C = (218.1, 343.8)
BOSS_HOLE_R = 7.7 * UNIT
BOSS_HOLE_DEPTH = 60.0 * UNIT

SIDE_HOLE_U = 138.5
SIDE_HOLE_Z = 71.4 * UNIT
SIDE_HOLE_R = 7.8 * UNIT

# toothed rib (arc band)
RIB_C = (-185.0, 558.6)
RIB_RO = 384.2          # outer (smooth) radius
RIB_RG = 372.0          # radius at tooth gaps
RIB_RT = 367.0          # radius at tooth tips
RIB_POCKET = 5.0 * UNIT # height of the teeth below the rib top
RIB_A0, RIB_A1 = -42.0, -14.0
TEETH = [(-35.0, -32.15), (-28.9, -26.5), (-23.1, -20.3)]
# rounded cap of the rib at the wall: start, arc mid, arc end, step point
RIB_CAP = [(117.6, 329.4), (111.6, 335.6), (113.2, 343.2), (116.6, 346.6)]

# groove around the lower lobe
GROOVE_Z0 = 9.3 * UNIT
GROOVE_Z1 = 13.0 * UNIT
GROOVE_D = 5.0 * UNIT
LOWER_INSET = 2.5 * UNIT
GROOVE_ZONE_V = 457.0     # groove / set-back run from here to the lobe tip

# clip profile
C_CEN = (190.5, 306.8)  # C-hole centre
C_R = 24.0
WALL_V0, WALL_V1 = 323.5, 344.5
WALL_U0 = 121.3
EAR_TOP_V = 327.5
EAR_INSET = 1.0         # clip profile sits slightly behind the plate edge
EAR_FILLET = 9.0        # plate corner fillet (ear uses EAR_FILLET - EAR_INSET)

# hypotenuse of the triangle plate
HYP_P = (179.2, 432.3)
HYP_Q = (240.4, 341.9)

LOBE_C = (135.5, 486.0)
LOBE_R = 21.7
LOBE_CORNER = (162.7, 458.5)  # sharp corner where the lobe meets the dent
CONC_C = (-20.7, 481.2)   # centre of the large concave edge


def P(p):
    u, v = p
    return ((u - U0) * UNIT, (V0 - v) * UNIT)


def add(a, b):
    return (a[0] + b[0], a[1] + b[1])


def sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def mul(a, s):
    return (a[0] * s, a[1] * s)


def norm(a):
    l = math.hypot(a[0], a[1])
    return (a[0] / l, a[1] / l)


def dot(a, b):
    return a[0] * b[0] + a[1] * b[1]


def on_circle(c, r, ang):
    a = math.radians(ang)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def ang_of(c, p):
    return math.degrees(math.atan2(p[1] - c[1], p[0] - c[0]))


def build(start, segs):
    """Build a closed wire workplane from drafting-unit segments."""
    wp = cq.Workplane("XY").moveTo(*P(start))
    cur = P(start)
    for s in segs:
        if s[0] == "L":
            wp = wp.lineTo(*P(s[1]))
            cur = P(s[1])
        elif s[0] == "A":
            wp = wp.threePointArc(P(s[1]), P(s[2]))
            cur = P(s[2])
        elif s[0] == "S":
            # interpolating spline, chord-length parametrised, with end
            # tangents (directions given in drafting units)
            pts = [P(q) for q in s[1]]
            allp = [cur] + pts
            par = [0.0]
            for a, b in zip(allp[:-1], allp[1:]):
                par.append(par[-1] + math.hypot(b[0] - a[0], b[1] - a[1]))
            length = par[-1]
            par = [p / length for p in par]
            tans = None
            if len(s) > 2 and s[2] is not None:
                t0, t1 = norm(s[2][0]), norm(s[2][1])
                tans = [(t0[0] * length, -t0[1] * length), (t1[0] * length, -t1[1] * length)]
            wp = wp.spline(pts, tangents=tans, parameters=par, scale=False, includeCurrent=True)
            cur = pts[-1]
    return wp.close()


def fillet_lines(p_corner, d1, d2, r, with_center=False):
    """Fillet between two rays leaving p_corner along d1 and d2."""
    d1 = norm(d1)
    d2 = norm(d2)
    cosang = dot(d1, d2)
    half = math.acos(max(-1.0, min(1.0, cosang))) / 2.0
    t = r / math.tan(half)
    p1 = add(p_corner, mul(d1, t))
    p2 = add(p_corner, mul(d2, t))
    bis = norm(add(d1, d2))
    cen = add(p_corner, mul(bis, r / math.sin(half)))
    mid = add(cen, mul(bis, -r))
    if with_center:
        return p1, mid, p2, cen
    return p1, mid, p2


def arc_points(c, r, a0, a1, n):
    """n interior points of the arc from angle a0 to a1 (degrees)."""
    return [on_circle(c, r, a0 + (a1 - a0) * (i + 1) / (n + 1)) for i in range(n)]


# ---------------------------------------------------------------------------
# derived geometry
# ---------------------------------------------------------------------------
HYP_D = norm(sub(HYP_Q, HYP_P))                 # up-right along hypotenuse
HYP_N = norm((-HYP_D[1], HYP_D[0]))
if dot(sub(BOSS_C, HYP_P), HYP_N) > 0:
    HYP_N = mul(HYP_N, -1.0)                    # outward normal
BOSS_RF = -dot(sub(BOSS_C, HYP_P), HYP_N)       # distance boss centre -> hypotenuse
BOSS_R = BOSS_RF - EAR_INSET                     # boss tangent to inset line
BOSS_T = add(BOSS_C, mul(HYP_N, BOSS_R))         # tangent point (ear)


def hyp_at_v(v, inset=0.0):
    s = (v - HYP_P[1]) / HYP_D[1]
    p = add(HYP_P, mul(HYP_D, s))
    if inset:
        # shift the line inwards, keep the same v
        p = add(p, mul(HYP_N, -inset))
        p = (p[0] + (HYP_D[0] / HYP_D[1]) * (v - p[1]), v)
    return p


def lobe_geometry():
    """Side line + lobe circle (joined smoothly) and the concave arc."""
    dlc = math.hypot(LOBE_C[0] - CONC_C[0], LOBE_C[1] - CONC_C[1])
    conc_r = dlc - LOBE_R
    tp = add(CONC_C, mul(norm(sub(LOBE_C, CONC_C)), conc_r))
    dc = sub(LOBE_CORNER, LOBE_C)
    dd = math.hypot(*dc)
    a_t = math.degrees(math.atan2(dc[1], dc[0])) + math.degrees(math.acos(LOBE_R / dd))
    a_l = ang_of(LOBE_C, tp)
    if a_l < a_t:
        a_l += 360.0
    return conc_r, tp, a_t, a_l


# ---------------------------------------------------------------------------
# tall extruded clip profile
# ---------------------------------------------------------------------------
def tall_profile():
    cu, cv = C_CEN
    c_top_v = cv - math.sqrt(C_R ** 2 - (200.0 - cu) ** 2)
    # convex fillet C-arc -> ear top line
    rf = 4.0
    fv = EAR_TOP_V + rf
    fu = cu + math.sqrt((C_R + rf) ** 2 - (fv - cv) ** 2)
    fc = (fu, fv)
    tc = add(C_CEN, mul(norm(sub(fc, C_CEN)), C_R))
    tl = (fu, EAR_TOP_V)
    fm = add(fc, mul(norm(add(norm(sub(tc, fc)), (0.0, -1.0))), rf))
    # ear corner fillet (top line / hypotenuse)
    corner = hyp_at_v(EAR_TOP_V, EAR_INSET)
    e1, em, e2, ec = fillet_lines(
        corner, (-1.0, 0.0), mul(HYP_D, -1.0), EAR_FILLET - EAR_INSET, with_center=True
    )
    # boss arc and fillet into wall front
    rw = 5.0
    bu, bv = BOSS_C
    wv = WALL_V1
    wfc_v = wv + rw
    wfc_u = bu - math.sqrt((BOSS_R + rw) ** 2 - (wfc_v - bv) ** 2)
    wfc = (wfc_u, wfc_v)
    wt_boss = add(BOSS_C, mul(norm(sub(wfc, BOSS_C)), BOSS_R))
    wt_line = (wfc_u, wv)
    wm = add(wfc, mul(norm(add(norm(sub(wt_boss, wfc)), (0.0, -1.0))), rw))
    a0 = ang_of(BOSS_C, BOSS_T)
    a1 = ang_of(BOSS_C, wt_boss)
    # ear outline (corner fillet -> flat -> boss) as one smooth curve
    rfe = EAR_FILLET - EAR_INSET
    fa0 = ang_of(ec, e1)
    fa1 = ang_of(ec, e2)
    # sample the hull (fillet arc, flat, boss arc) at even arc-length steps
    l_f = math.radians(abs(fa1 - fa0)) * rfe
    l_s = math.hypot(*sub(BOSS_T, e2))
    l_b = math.radians(abs(a1 - a0)) * BOSS_R
    total = l_f + l_s + l_b
    n_ear = 12
    ear_pts = []
    for i in range(1, n_ear + 1):
        d = total * i / n_ear
        if d <= l_f:
            ear_pts.append(on_circle(ec, rfe, fa0 + (fa1 - fa0) * d / l_f))
        elif d <= l_f + l_s:
            ear_pts.append(add(e2, mul(sub(BOSS_T, e2), (d - l_f) / l_s)))
        else:
            ear_pts.append(on_circle(BOSS_C, BOSS_R, a0 + (a1 - a0) * min(1.0, (d - l_f - l_s) / l_b)))
    t_ear1 = (-math.sin(math.radians(a1)), math.cos(math.radians(a1)))

    k = 0.2929
    segs = [
        ("L", (125.3, 275.3)),
        ("A", (125.3 + 4 * k, 271.3 + 4 * k), (129.3, 271.3)),
        ("L", (194.6, 271.3)),
        ("L", (217.0, 277.3)),
        ("A", (218.8, 278.4), (219.2, 280.0)),
        ("L", (219.2, 287.3)),
        ("A", (219.2 - 1.5 * k, 288.8 - 1.5 * k), (217.7, 288.8)),
        ("L", (208.0, 288.8)),
        ("L", (208.0, 292.2)),
        ("A", (208.0 - 2 * k, 294.2 - 2 * k), (206.0, 294.2)),
        ("L", (202.0, 294.2)),
        ("A", (200.0 + 2 * k, 294.2 - 2 * k), (200.0, 292.2)),
        ("L", (200.0, c_top_v)),
        ("A", (cu - C_R, cv), tc),
        ("A", fm, tl),
        ("L", e1),
        ("S", ear_pts, ((1.0, 0.0), t_ear1)),
        ("A", wm, wt_line),
        ("L", (WALL_U0 + 3.0, WALL_V1)),
        ("A", (WALL_U0 + 3 * k, WALL_V1 - 3 * k), (WALL_U0, WALL_V1 - 3.0)),
        ("L", (WALL_U0, WALL_V0 + 3.0)),
        ("A", (WALL_U0 + 3 * k, WALL_V0 + 3 * k), (WALL_U0 + 3.0, WALL_V0)),
        ("L", (152.3, WALL_V0)),
        ("A", (152.3 + 3 * 0.7071, WALL_V0 - 3.0 + 3 * 0.7071), (155.3, WALL_V0 - 3.0)),
        ("L", (155.3, 312.0)),
        ("A", (156.3, 297.5), (160.5, 282.5)),
        ("L", (129.3, 282.5)),
        ("A", (125.3 + 4 * k, 282.5 - 4 * k), (125.3, 278.5)),
    ]
    return build((125.3, 278.5), segs).extrude(H_TALL)


# ---------------------------------------------------------------------------
# base plate outline (fan lever + triangle plate)
# ---------------------------------------------------------------------------
def base_segments():
    # rib end cap at the triangle tip
    r_cap = 6.0
    n_in = mul(HYP_N, -1.0)
    cap_c_v = 440.3 - r_cap
    lv = cap_c_v - r_cap * n_in[1]
    lp = hyp_at_v(lv)
    cap_c = add(lp, mul(n_in, r_cap))
    cap_mid = (cap_c[0], cap_c[1] + r_cap)
    cap_end = on_circle(cap_c, r_cap, 150.0)

    # plate top-right corner
    top_v = EAR_TOP_V + 0.5
    corner = hyp_at_v(top_v)
    p1, pm, p2 = fillet_lines(corner, (-1.0, 0.0), mul(HYP_D, -1.0), EAR_FILLET)

    # lobe: side line from the corner, tangent onto the lobe circle, which in
    # turn runs tangentially into the large concave arc
    conc_r, tp, a_t, a_l = lobe_geometry()
    lobe_right = on_circle(LOBE_C, LOBE_R, a_t)
    lobe_dir = norm(sub(lobe_right, LOBE_CORNER))
    lobe_pts = (
        [mul(add(LOBE_CORNER, lobe_right), 0.5), lobe_right]
        + arc_points(LOBE_C, LOBE_R, a_t, a_l, 5)
        + [tp]
    )
    t_lobe1 = (-math.sin(math.radians(a_l)), math.cos(math.radians(a_l)))
    a_tp = ang_of(CONC_C, tp)
    a_top = -57.6
    conc_mid = on_circle(CONC_C, conc_r, (a_tp + a_top) / 2.0)
    conc_end = on_circle(CONC_C, conc_r, a_top)
    t_start = (math.sin(math.radians(a_top)), -math.cos(math.radians(a_top)))

    wiggle = [
        (47.9, 367.4), (41.8, 373.9), (36.0, 375.8), (30.6, 373.1),
        (28.9, 368.5), (32.3, 362.7), (32.9, 358.3), (28.0, 354.0),
        (22.0, 351.9),
    ]
    segs = [
        ("L", (208.0, 336.0)),
        ("L", (208.0, top_v)),
        ("L", p1),
        ("A", pm, p2),
        ("L", lp),
        ("A", cap_mid, cap_end),
        ("L", (157.2, 447.8)),
        ("A", (155.0, 451.8), (158.0, 455.0)),
        ("L", LOBE_CORNER),
        ("S", lobe_pts, (lobe_dir, t_lobe1)),
        ("A", conc_mid, conc_end),
        ("S", wiggle, (t_start, (-0.96, -0.28))),
        ("A", (18.6, 346.5), (24.0, 341.1)),
        ("A", (85.0, 339.0), (111.0, 334.3)),
        ("A", (113.6, 331.0), (117.6, 329.4)),
        ("L", (121.5, 329.0)),
    ]
    return (121.5, 336.0), segs


def base_prism(h):
    st, segs = base_segments()
    return build(st, segs).extrude(h)


# ---------------------------------------------------------------------------
# toothed rib
# ---------------------------------------------------------------------------
def rib_band(z0, z1, teeth=True):
    """Arc-shaped rib: smooth outer edge, square teeth on the inner edge and a
    rounded cap where it runs into the wall (teeth=False gives the plain band
    at the tooth-root radius carrying the teeth)."""
    c = RIB_C
    a_wall = -37.0                                   # outer edge enters the wall
    start = on_circle(c, RIB_RO, RIB_A1)
    segs = [
        ("A", on_circle(c, RIB_RO, (RIB_A1 + a_wall) / 2), on_circle(c, RIB_RO, a_wall)),
        ("L", RIB_CAP[0]),
        ("A", RIB_CAP[1], RIB_CAP[2]),
        ("L", RIB_CAP[3]),
    ]
    a_cap = ang_of(c, RIB_CAP[3])
    r_cap = math.hypot(*sub(RIB_CAP[3], c))
    # inner edge from the cap down to A1: tooth / gap alternation
    edges = []
    cur = a_cap
    for (t0, t1) in (TEETH if teeth else []):
        if t0 > cur + 0.3:
            edges.append((RIB_RG, cur, t0))
        else:
            t0 = cur
        edges.append((RIB_RT, t0, t1))
        cur = t1
    if cur < RIB_A1 - 0.01:
        edges.append((RIB_RG, cur, RIB_A1))
    prev_r = r_cap
    for (r, a_from, a_to) in edges:
        if abs(r - prev_r) > 1e-6:
            segs.append(("L", on_circle(c, r, a_from)))
        segs.append(("A", on_circle(c, r, (a_from + a_to) / 2), on_circle(c, r, a_to)))
        prev_r = r
    return build(start, segs).extrude(z1 - z0).translate((0, 0, z0))


# ---------------------------------------------------------------------------
# assembly of features
# ---------------------------------------------------------------------------
base = base_prism(H_PLATE)
rib = (
    rib_band(0.0, H_RIB - RIB_POCKET + 0.01, teeth=False)
    .union(rib_band(H_RIB - RIB_POCKET, H_RIB, teeth=True))
    .intersect(base_prism(H_RIB))
)
tall = tall_profile()

body = base.union(rib).union(tall)

# pins with chamfered tops (cylinder seam turned to the back-right)
for pc in (PIN1, PIN2):
    px, py = P(pc)
    pin_plane = cq.Plane(origin=(px, py, H_PLATE - 0.01), xDir=(1, 1, 0), normal=(0, 0, 1))
    pin = (
        cq.Workplane(pin_plane)
        .circle(PIN_R)
        .extrude(H_PIN - H_PLATE + 0.01)
        .faces(">Z")
        .edges()
        .chamfer(PIN_CHAMFER)
    )
    body = body.union(pin)

# groove around the lower lobe and slightly set-back lower half of the lobe
zu0, zv0 = P((LOBE_C[0] - 40.0, GROOVE_ZONE_V))
zu1, zv1 = P((LOBE_C[0] + 40.0, LOBE_C[1] + 40.0))


def lobe_inner(depth):
    """Lobe outline offset inwards by `depth`, closed through the interior."""
    conc_r, tp, a_t, a_l = lobe_geometry()
    r_in = LOBE_R - depth
    lr = on_circle(LOBE_C, r_in, a_t)
    sd = norm(sub(LOBE_CORNER, on_circle(LOBE_C, LOBE_R, a_t)))   # side, upwards
    top_v = GROOVE_ZONE_V - 8.0
    s_top = add(lr, mul(sd, (top_v - lr[1]) / sd[1]))
    rc = conc_r + depth
    a_tp = ang_of(CONC_C, tp)
    a_top = -math.degrees(math.asin((CONC_C[1] - top_v) / rc))
    c_top = on_circle(CONC_C, rc, a_top)
    pts = (
        [mul(add(s_top, lr), 0.5), lr]
        + arc_points(LOBE_C, r_in, a_t, a_l, 5)
        + [on_circle(LOBE_C, r_in, a_l)]
    )
    t0 = mul(sd, -1.0)
    t1 = (-math.sin(math.radians(a_l)), math.cos(math.radians(a_l)))
    segs = [
        ("S", pts, (t0, t1)),
        ("A", on_circle(CONC_C, rc, (a_tp + a_top) / 2.0), c_top),
    ]
    return build(s_top, segs)


def edge_ring(depth, z0, z1):
    inner = lobe_inner(depth / UNIT).extrude(z1 - z0 + 2.0).translate((0, 0, z0 - 1.0))
    slab = (
        cq.Workplane("XY")
        .center((zu0 + zu1) / 2, (zv0 + zv1) / 2)
        .rect(abs(zu1 - zu0), abs(zv1 - zv0))
        .extrude(z1 - z0)
        .translate((0, 0, z0))
    )
    return slab.cut(inner)


body = body.cut(edge_ring(GROOVE_D, GROOVE_Z0, GROOVE_Z1))
body = body.cut(edge_ring(LOWER_INSET, -0.5, GROOVE_Z0 + 0.01))

# holes
tri_hole = (
    cq.Workplane("XY")
    .center(*P(TRI_HOLE))
    .circle(TRI_HOLE_R)
    .extrude(H_RIB)
    .translate((0, 0, -1))
)
body = body.cut(tri_hole)
# small countersink of the triangle hole on the underside
body = body.cut(
    cq.Workplane("XY")
    .add(
        cq.Solid.makeCone(
            TRI_HOLE_R + TRI_HOLE_CSK,
            0.0,
            TRI_HOLE_R + TRI_HOLE_CSK,
            cq.Vector(*P(TRI_HOLE), 0.0),
            cq.Vector(0, 0, 1),
        )
    )
)
bx, by = P(BOSS_C)
boss_plane = cq.Plane(origin=(bx, by, H_TALL - BOSS_HOLE_DEPTH), xDir=(1, -1, 0), normal=(0, 0, 1))
body = body.cut(cq.Workplane(boss_plane).circle(BOSS_HOLE_R).extrude(BOSS_HOLE_DEPTH + 1))
sx, sy = P((SIDE_HOLE_U, WALL_V0 - 5))
body = body.cut(
    cq.Workplane("XZ", origin=(0, sy, 0))
    .center(sx, SIDE_HOLE_Z)
    .circle(SIDE_HOLE_R)
    .extrude(40 * UNIT)
)

# narrow slit in the underside of the lower lobe
sl0 = P((SLIT_U0, SLIT_V))
sl1 = P((SLIT_U1, SLIT_V))
body = body.cut(
    cq.Workplane("XY")
    .center((sl0[0] + sl1[0]) / 2, sl0[1])
    .slot2D(abs(sl1[0] - sl0[0]), SLIT_W)
    .extrude(SLIT_H)
    .translate((0, 0, -0.01))
)

# chamfer along the bottom edge of the hypotenuse face
hp0 = P(hyp_at_v(437.0))
hp1 = P(hyp_at_v(341.0))
hd = norm(sub(hp1, hp0))
hn = (hd[1], -hd[0])
if dot(sub(P(TRI_HOLE), hp0), hn) > 0:
    hn = mul(hn, -1.0)          # outward normal of the hypotenuse in XY
c = BOTTOM_CHAMFER
p_out = add(hp0, mul(hn, 1.0))
p_in = add(hp0, mul(hn, -c))
tri = cq.Wire.makePolygon(
    [
        cq.Vector(p_out[0], p_out[1], -1.0),
        cq.Vector(p_in[0], p_in[1], -1.0),
        cq.Vector(p_in[0], p_in[1], 0.0),
        cq.Vector(p_out[0], p_out[1], c + 1.0),
    ],
    close=True,
)
span = math.hypot(hp1[0] - hp0[0], hp1[1] - hp0[1])
cutter = cq.Solid.extrudeLinear(cq.Face.makeFromWires(tri), cq.Vector(hd[0] * span, hd[1] * span, 0))
body = body.cut(cq.Workplane("XY").add(cutter))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
